import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
WING_ANGLE = 7.7          # each half rotated by this angle (deg)
TL_X, TL_Y = -152.0, 67.2  # virtual back-outer corner of the left wing
WING_DEPTH = 116.4        # depth of a wing, measured along its own axis
CENTER_HALF_W = 14.0      # half width of the back centre (usb) section
CENTER_RECESS = 0.9       # the centre section sits this much forward of the wing walls
NOTCH_FLAT_HALF = 9.2     # half length of the flat in the front notch
NOTCH_FLAT_Y = -57.8      # y of the flat in the front notch
NOTCH_SLANT = 17.7        # slope of the notch side segments (deg)
CORNER_CH = 5.0           # vertical chamfer on the four outer corners

H = 15.0                  # overall height
FLOOR_T = 2.5             # floor thickness
WALL_T = 5.4              # wall thickness at the top
TOP_CH = 3.3              # 45 deg chamfer on the outer top edge
LEDGE_W = 3.5             # inner ledge width
LEDGE_H = 3.0             # inner ledge height above floor
RABBET_W = 0.3            # small step in the upper inner wall face
RABBET_D = 3.3            # depth of that step from the top

BOSS_D = 9.5
BOSS_H = 3.0              # above the floor
HEX_AF = 5.6              # hex pocket across flats
HEX_DEPTH = 2.0
HOLE_D = 3.0

PORT_NOTCH_W = 16.0       # outer recess for the usb plug
PORT_NOTCH_H = 9.5
PORT_NOTCH_D = 3.5
PORT_W = 11.0             # usb opening
PORT_H = 4.4
PORT_TOP = 3.3            # opening top below wall top

FOOT_D = 7.0              # round recesses for rubber feet ...
FOOT_SLOT_L = 16.0        # ... with a narrow slot through them
FOOT_SLOT_W = 1.4
FOOT_DEPTH = 1.0
SLOT_L = 16.5
SLOT_W = 1.5
SLOT_DEPTH = 1.0

# ---------------- outline ----------------
a = math.radians(WING_ANGLE)
u = (math.cos(a), -math.sin(a))   # left wing long axis
v = (math.sin(a), math.cos(a))    # left wing depth axis

TL = (TL_X, TL_Y)
BL = (TL_X - WING_DEPTH * v[0], TL_Y - WING_DEPTH * v[1])

# back edge reaches the centre section, which is set forward by CENTER_RECESS
t_back = (-CENTER_HALF_W - TL[0]) / u[0]
T1 = (-CENTER_HALF_W, TL[1] + t_back * u[1])
BACK_FLAT_Y = T1[1] - CENTER_RECESS
T0 = (-CENTER_HALF_W, BACK_FLAT_Y)

# front edge meets the notch slant
b = math.radians(NOTCH_SLANT)
B2 = (-NOTCH_FLAT_HALF, NOTCH_FLAT_Y)
# front line: BL + s*u ; slant line: B2 + r*(-cos b, -sin b)
dx, dy = B2[0] - BL[0], B2[1] - BL[1]
w = (-math.cos(b), -math.sin(b))
det = u[0] * (-w[1]) - u[1] * (-w[0])
s = (dx * (-w[1]) - dy * (-w[0])) / det
B1 = (BL[0] + s * u[0], BL[1] + s * u[1])


def mir(p):
    return (-p[0], p[1])


def chamfer_corner(prev, corner, nxt, c):
    """replace a sharp corner by two points c away along each edge"""
    def toward(p, q, d):
        L = math.hypot(q[0] - p[0], q[1] - p[1])
        return (p[0] + (q[0] - p[0]) * d / L, p[1] + (q[1] - p[1]) * d / L)
    return [toward(corner, prev, c), toward(corner, nxt, c)]


raw = [BL, B1, B2, mir(B2), mir(B1), mir(BL), mir(TL), mir(T1), mir(T0), T0, T1, TL]
chamfered = {0, 5, 6, 11}
pts = []
n = len(raw)
for i, p in enumerate(raw):
    if i in chamfered:
        pts += chamfer_corner(raw[i - 1], p, raw[(i + 1) % n], CORNER_CH)
    else:
        pts.append(p)

outer_wire = cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True)


def offset_face(d, z0, z1):
    wr = outer_wire.offset2D(-d, kind="intersection")[0] if d > 0 else outer_wire
    f = cq.Face.makeFromWires(wr)
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(f, cq.Vector(0, 0, z1 - z0))).translate((0, 0, z0))


# ---------------- body ----------------
body = cq.Workplane("XY").add(cq.Solid.extrudeLinear(cq.Face.makeFromWires(outer_wire), cq.Vector(0, 0, H)))
body = body.faces(">Z").edges().chamfer(TOP_CH)

# cavity above the ledge, ledge cavity, rabbet
body = body.cut(offset_face(WALL_T, FLOOR_T + LEDGE_H, H + 1))
body = body.cut(offset_face(WALL_T + LEDGE_W, FLOOR_T, FLOOR_T + LEDGE_H + 0.01))
body = body.cut(offset_face(WALL_T - RABBET_W, H - RABBET_D, H + 1))

# ---------------- bosses ----------------
boss_pts = [
    (-123.6, 30.2), (-130.3, -19.6),
    (-7.5, -24.1), (-19.9, -35.2),
    (-7.4, 38.2),
]
boss_pts = boss_pts + [mir(p) for p in boss_pts]

bosses = (
    cq.Workplane("XY").workplane(offset=FLOOR_T - 0.5)
    .pushPoints(boss_pts).circle(BOSS_D / 2).extrude(BOSS_H + 0.5)
)
body = body.union(bosses)
hexes = (
    cq.Workplane("XY").workplane(offset=FLOOR_T + BOSS_H - HEX_DEPTH)
    .pushPoints(boss_pts).polygon(6, HEX_AF / math.cos(math.pi / 6)).extrude(HEX_DEPTH + 5)
)
body = body.cut(hexes)
holes = cq.Workplane("XY").workplane(offset=-1).pushPoints(boss_pts).circle(HOLE_D / 2).extrude(H + 2)
body = body.cut(holes)

# ---------------- usb port in the back flat ----------------
notch = (
    cq.Workplane("XY")
    .center(0, BACK_FLAT_Y - PORT_NOTCH_D / 2 + 0.5)
    .rect(PORT_NOTCH_W, PORT_NOTCH_D + 1)
    .extrude(PORT_NOTCH_H + 1)
    .translate((0, 0, H - PORT_NOTCH_H))
)
body = body.cut(notch)
port_z0 = H - PORT_TOP - PORT_H
port = (
    cq.Workplane("XY")
    .center(0, BACK_FLAT_Y - 10)
    .rect(PORT_W, 20.5)
    .extrude(PORT_H)
    .translate((0, 0, port_z0))
)
body = body.cut(port)

# ---------------- underside: feet recesses and slots ----------------
feet = [(-144.0, -31.0), (-135.3, 44.4)]
feet = feet + [mir(p) for p in feet]
for fx, fy in feet:
    ft = cq.Workplane("XY").circle(FOOT_D / 2).extrude(FOOT_DEPTH)
    ft = ft.union(cq.Workplane("XY").slot2D(FOOT_SLOT_L, FOOT_SLOT_W).extrude(FOOT_DEPTH))
    ft = ft.translate((fx, fy, -0.01))
    body = body.cut(ft)

for sx, sy in [(-37.5, -43.6), (0.0, -19.4), (37.5, -43.6)]:
    sl = (cq.Workplane("XY").slot2D(SLOT_L, SLOT_W, angle=90).extrude(SLOT_DEPTH)
          .translate((sx, sy, -0.01)))
    body = body.cut(sl)

result = body
